"""Flexure clamp block: low front mounting body, raised rear clamp block with a
rounded hinge barrel, vertical bore with a ledge, flexure slit + relief hole,
side window into the bore, clamp-screw holes along X and a cross-pin hole along Y."""
import math

import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 50.5            # overall width (X)
D = 59.4            # overall depth (Y)
H1 = 16.8           # height of the low front body
H2 = 20.4           # top face of the raised clamp block

# rear clamp block footprint
RX0 = 2.4           # left face of the rear block
RX1 = 32.5          # right face of the rear block
RY0 = 34.85         # front face of the raised part
NOTCH_X = 5.25      # rear-left notch: the barrel section starts here
NOTCH_Y = 51.15     # rear-left notch front face

# rounded hinge barrel along the rear top edge (axis along X)
BAR_R = 4.0
BAR_Y = D - BAR_R
BAR_Z = H1

# concave sweeps on both sides (front body -> rear block): equal radius,
# each tangent to a rear-block side face at the same Y
ARC_R = 22.7
ARC_CY = 37.3

# flexure slit + relief hole
REL_X = 26.4        # also the centreline of the mounting-hole pattern
REL_Y = 25.25
REL_R = 4.25
SLIT_W = 1.2
SLIT_X0 = REL_X - REL_R     # slit runs tangent to the relief hole

# counterbored mounting holes through the front body
MH_Y = 6.65
MH_DX = 18.475      # half spacing about the centreline
MH_D = 4.0
MH_CB_D = 7.5
MH_CB_H = 9.0

# main vertical bore (counterbore on top, ledge, through bore)
BORE_X = 14.2
BORE_Y = 45.6
BORE_D = 10.6
BORE_CB_D = 12.15
BORE_CB_H = 4.6

# blind counterbored hole in the flexure arm (opens into the slit)
SH_X = 26.5
SH_D = 3.7
SH_CB_D = 7.3
SH_CB_H = 4.5
SH_BOTTOM_Z = 13.2  # stops above the side window

# clamp screw holes along X through the barrel section
XH_Y = 55.45
XH_Z = (16.75, 3.1)
XH_D = 3.85

# cross pin hole along Y (grazes the bore), counterbored at the front
YH_X = 19.25
YH_Z = 9.0
YH_D = 2.5
YH_CB_D = 5.1
YH_CB_H = 5.0

# rectangular side window in the +X face, running into the bore
WIN_Y0, WIN_Y1 = 38.95, 52.2
WIN_Z0, WIN_Z1 = 5.85, 12.0
WIN_XEND = 16.2

# shallow obround pocket in the far wall of the bore, facing the window
POCK_L = 6.2        # length along Y
POCK_H = 3.0        # height along Z
POCK_Z = 8.9
POCK_XBOT = 8.4     # pocket floor X

BIG = 100.0         # generic "through" length


# ---------------- helpers ----------------
def arc_mid(cx, cy, r, a0, a1):
    """point on a circle half way between polar angles a0 and a1"""
    a = 0.5 * (a0 + a1)
    return (cx + r * math.cos(a), cy + r * math.sin(a))


def zcyl(x, y, d, z0, h):
    return cq.Workplane("XY").workplane(offset=z0).center(x, y).circle(d / 2.0).extrude(h)


def box(x0, x1, y0, y1, z0, z1):
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False).translate((x0, y0, z0))


# ---------------- base body: low front block + rear footprint ----------------
rcx = RX1 + ARC_R                                   # right sweep centre
r_y_end = ARC_CY - math.sqrt(ARC_R ** 2 - (rcx - W) ** 2)
r_a0 = math.atan2(r_y_end - ARC_CY, W - rcx) % (2 * math.pi)
r_mid = arc_mid(rcx, ARC_CY, ARC_R, r_a0, math.pi)

lcx = RX0 - ARC_R                                   # left sweep centre
l_y_end = ARC_CY - math.sqrt(ARC_R ** 2 - lcx ** 2)
l_a1 = math.atan2(l_y_end - ARC_CY, -lcx)
l_mid = arc_mid(lcx, ARC_CY, ARC_R, 0.0, l_a1)

base = (
    cq.Workplane("XY")
    .moveTo(0, 0)
    .lineTo(W, 0)
    .lineTo(W, r_y_end)
    .threePointArc(r_mid, (RX1, ARC_CY))
    .lineTo(RX1, D)
    .lineTo(NOTCH_X, D)
    .lineTo(NOTCH_X, NOTCH_Y)
    .lineTo(RX0, NOTCH_Y)
    .lineTo(RX0, ARC_CY)
    .threePointArc(l_mid, (0, l_y_end))
    .close()
    .extrude(H1)
)

# ---------------- raised rear block with the hinge barrel (YZ profile extruded along X) ----------------
yb = math.sqrt(BAR_R ** 2 - (H2 - BAR_Z) ** 2)       # barrel / flat-top intersection offset
top_a = math.atan2(H2 - BAR_Z, -yb)                  # polar angle of that intersection
rear = (
    cq.Workplane("YZ", origin=(RX0, 0, 0))
    .moveTo(RY0, 0)
    .lineTo(D, 0)
    .lineTo(D, BAR_Z)
    .threePointArc(arc_mid(BAR_Y, BAR_Z, BAR_R, 0.0, math.pi / 2), (BAR_Y, BAR_Z + BAR_R))
    .threePointArc(arc_mid(BAR_Y, BAR_Z, BAR_R, math.pi / 2, top_a), (BAR_Y - yb, H2))
    .lineTo(RY0, H2)
    .close()
    .extrude(RX1 - RX0)
)
body = base.union(rear)

# rear-left notch: the barrel section is narrower than the clamp block
body = body.cut(box(RX0 - 2, NOTCH_X, NOTCH_Y, D + 2, -5, 30))

# ---------------- flexure slit + relief hole ----------------
body = body.cut(box(SLIT_X0, SLIT_X0 + SLIT_W, REL_Y, D + 2, -5, 30))
body = body.cut(zcyl(REL_X, REL_Y, 2 * REL_R, -5, BIG))

# ---------------- counterbored mounting holes (from the top of the front body) ----------------
for mx in (REL_X - MH_DX, REL_X + MH_DX):
    body = body.cut(zcyl(mx, MH_Y, MH_D, -5, BIG))
    body = body.cut(zcyl(mx, MH_Y, MH_CB_D, H1 - MH_CB_H, BIG))

# ---------------- main bore with a ledge ----------------
body = body.cut(zcyl(BORE_X, BORE_Y, BORE_D, -5, BIG))
body = body.cut(zcyl(BORE_X, BORE_Y, BORE_CB_D, H2 - BORE_CB_H, BIG))

# ---------------- side window running from the +X face into the bore ----------------
body = body.cut(box(WIN_XEND, RX1 + 2, WIN_Y0, WIN_Y1, WIN_Z0, WIN_Z1))

# ---------------- obround pocket opposite the window ----------------
pocket = (
    cq.Workplane("YZ", origin=(POCK_XBOT, 0, 0))
    .center(BORE_Y, POCK_Z)
    .slot2D(POCK_L, POCK_H, 0)
    .extrude(BORE_X - POCK_XBOT)
)
body = body.cut(pocket)

# ---------------- blind counterbored hole in the flexure arm ----------------
body = body.cut(zcyl(SH_X, BORE_Y, SH_D, SH_BOTTOM_Z, BIG))
body = body.cut(zcyl(SH_X, BORE_Y, SH_CB_D, H2 - SH_CB_H, BIG))

# ---------------- clamp screw holes along X through the barrel section ----------------
for z in XH_Z:
    xh = cq.Workplane("YZ", origin=(-5, 0, 0)).center(XH_Y, z).circle(XH_D / 2.0).extrude(W + 10)
    body = body.cut(xh)

# ---------------- cross pin hole along Y, counterbored from the front ----------------
yh = cq.Workplane("XZ", origin=(0, -5, 0)).center(YH_X, YH_Z).circle(YH_D / 2.0).extrude(-(D + 10))
yh_cb = cq.Workplane("XZ", origin=(0, -5, 0)).center(YH_X, YH_Z).circle(YH_CB_D / 2.0).extrude(-(YH_CB_H + 5))
body = body.cut(yh).cut(yh_cb)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
